import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 95.0            # overall width (X)
D = 84.5            # overall depth (Y); front of base at Y=0, back at Y=D
T = 25.6            # wall thickness (Y)
H_BASE = 15.3       # base plate thickness
H_MID = 26.7        # height of the middle (low) part of the wall
UP_W = 25.3         # upright width (X)
HOLE_OFF = 9.7      # upright hole centre from the outer side face
HOLE_Z = 44.4       # upright hole centre height
HOLE_D = 11.1       # upright hole diameter
ARC_R = UP_W - HOLE_OFF   # rounded top of the uprights (tangent to inner face)

BAR_HW = 39.5       # half width of the front bar
TAPER_L = 27.3      # length (Y) of the tapered transition bar -> wall

OPEN_BACK_HW = 23.7   # trapezoid window half width at the wall
OPEN_FRONT_HW = 15.5  # trapezoid window half width at its front edge
OPEN_L = 27.3         # trapezoid window length (Y)

GROOVE_Y = 15.6     # groove axis distance from the front face
GROOVE_R = 10.3     # main groove radius
GROOVE_HL = 34.0    # main groove half length
END_R = 5.5         # end groove radius (runs out through both ends)

NOTCH_X = [-28.6, -8.2, 8.2, 28.6]
NOTCH_W = 5.8
NOTCH_Y0 = 24.6
NOTCH_Y1 = 26.6

BACK_SAG = 10.8     # depth of the concave cut in the back of the middle wall

XHOLE_D = 7.8       # cross hole (X axis) low in the wall
XHOLE_Z = 9.0
XHOLE_FROM_BACK = 13.2

NUT_W = 8.0         # nut trap slot crossing the cross hole
NUT_Z0 = 2.5
NUT_Z1 = 16.2
NUT_DEPTH = 18.0    # measured from the back face

VHOLE_D = 6.6       # blind holes up into the uprights from below
VHOLE_FROM_BACK = 4.6
VHOLE_DEPTH = HOLE_Z  # runs up into the upright cross hole

TAB_W = 23.8        # slotted tab width (X), flush with the outer face
TAB_R = 10.6        # tab rounded top radius
TAB_CZ = 71.8       # tab top arc centre height
TAB_Z0 = 52.6       # height where the tab taper reaches full wall thickness
SLOT_R = 4.5
SLOT_Z0 = 54.3      # slot lower arc centre
SLOT_Z1 = 71.7      # slot upper arc centre
LEDGE_R = 9.0       # shallow counter recess around the slot (inner face)

# ---------------- derived ----------------
Y_WF = D - T        # wall front plane
Y_WC = D - T / 2.0  # wall centre plane
XL = -W / 2.0
XR = W / 2.0


# ---------------- base plate (top-view outline with straight taper) -------
bw = (
    cq.Workplane("XY")
    .polyline([
        (XL, D), (XR, D), (XR, Y_WF), (BAR_HW, Y_WF - TAPER_L), (BAR_HW, 0.0),
        (-BAR_HW, 0.0), (-BAR_HW, Y_WF - TAPER_L), (XL, Y_WF),
    ])
    .close()
)
base = bw.extrude(H_BASE)

# ---------------- wall with two rounded uprights (front-view profile) ----
xh = XR - HOLE_OFF
z_out = HOLE_Z + math.sqrt(ARC_R ** 2 - HOLE_OFF ** 2)
a_mid = math.atan2(z_out - HOLE_Z, HOLE_OFF)
a_m = (a_mid + math.pi) / 2.0
wall = (
    cq.Workplane("XZ", origin=(0, Y_WF, 0))
    .moveTo(XL, 0)
    .lineTo(XR, 0)
    .lineTo(XR, z_out)
    .threePointArc((xh + ARC_R * math.cos(a_m), HOLE_Z + ARC_R * math.sin(a_m)),
                   (XR - UP_W, HOLE_Z))
    .lineTo(XR - UP_W, H_MID)
    .lineTo(XL + UP_W, H_MID)
    .lineTo(XL + UP_W, HOLE_Z)
    .threePointArc((-xh - ARC_R * math.cos(a_m), HOLE_Z + ARC_R * math.sin(a_m)),
                   (XL, z_out))
    .close()
    .extrude(-T)
)

# ---------------- slotted tab on the left upright (side-view profile) ----
half_t = T / 2.0


def tangent_point(px, pz, cx, cz, r, side):
    dx, dz = px - cx, pz - cz
    d = math.hypot(dx, dz)
    phi = math.atan2(dz, dx)
    al = math.acos(r / d)
    a = phi + al if side > 0 else phi - al
    return (cx + r * math.cos(a), cz + r * math.sin(a))


tp_r = tangent_point(Y_WC + half_t, TAB_Z0, Y_WC, TAB_CZ, TAB_R, +1)
tp_l = tangent_point(Y_WC - half_t, TAB_Z0, Y_WC, TAB_CZ, TAB_R, -1)
tab = (
    cq.Workplane("YZ", origin=(XL, 0, 0))
    .moveTo(Y_WC - half_t, TAB_Z0 - 8.0)
    .lineTo(Y_WC + half_t, TAB_Z0 - 8.0)
    .lineTo(Y_WC + half_t, TAB_Z0)
    .lineTo(*tp_r)
    .threePointArc((Y_WC, TAB_CZ + TAB_R), tp_l)
    .lineTo(Y_WC - half_t, TAB_Z0)
    .close()
    .extrude(TAB_W)
)

body = base.union(wall).union(tab)

# ---------------- cuts ----------------
cuts = []

# upright cross holes (Y axis)
for s in (-1, 1):
    cuts.append(
        cq.Workplane("XZ", origin=(0, D + 1, 0))
        .center(s * xh, HOLE_Z)
        .circle(HOLE_D / 2.0)
        .extrude(T + 2)
    )

# concave cut in the back of the middle wall (vertical cylinder)
chord_h = W / 2.0 - UP_W
back_r = (chord_h ** 2 + BACK_SAG ** 2) / (2 * BACK_SAG)
cuts.append(
    cq.Workplane("XY", origin=(0, D + back_r - BACK_SAG, -1))
    .circle(back_r)
    .extrude(H_MID + 2)
)

# trapezoid window through the base in front of the wall
cuts.append(
    cq.Workplane("XY", origin=(0, 0, -1))
    .polyline([
        (-OPEN_BACK_HW, Y_WF),
        (OPEN_BACK_HW, Y_WF),
        (OPEN_FRONT_HW, Y_WF - OPEN_L),
        (-OPEN_FRONT_HW, Y_WF - OPEN_L),
    ])
    .close()
    .extrude(H_BASE + 2)
)

# main groove and through end groove (X axis)
cuts.append(
    cq.Workplane("YZ", origin=(-GROOVE_HL, 0, 0))
    .center(GROOVE_Y, H_BASE)
    .circle(GROOVE_R)
    .extrude(2 * GROOVE_HL)
)
cuts.append(
    cq.Workplane("YZ", origin=(-W, 0, 0))
    .center(GROOVE_Y, H_BASE)
    .circle(END_R)
    .extrude(2 * W)
)

# small through notches along the back edge of the groove
for nx in NOTCH_X:
    cuts.append(
        cq.Workplane("XY")
        .box(NOTCH_W, NOTCH_Y1 - NOTCH_Y0, H_BASE + 2, centered=(True, False, False))
        .translate((nx, NOTCH_Y0, -1))
    )

# cross hole along X low in the wall
cuts.append(
    cq.Workplane("YZ", origin=(-W, 0, 0))
    .center(D - XHOLE_FROM_BACK, XHOLE_Z)
    .circle(XHOLE_D / 2.0)
    .extrude(2 * W)
)

# nut trap slot crossing the cross hole, opened from the concave back
cuts.append(
    cq.Workplane("XY")
    .box(NUT_W, NUT_DEPTH + 5, NUT_Z1 - NUT_Z0, centered=(True, False, False))
    .translate((0, D - NUT_DEPTH, NUT_Z0))
)

# blind holes up into the uprights from the underside
for s in (-1, 1):
    cuts.append(
        cq.Workplane("XY", origin=(0, 0, -1))
        .center(s * xh, D - VHOLE_FROM_BACK)
        .circle(VHOLE_D / 2.0)
        .extrude(VHOLE_DEPTH + 1)
    )

# slot through the tab (X axis)
cuts.append(
    cq.Workplane("YZ", origin=(XL - 1, 0, 0))
    .center(Y_WC, (SLOT_Z0 + SLOT_Z1) / 2.0)
    .slot2D(SLOT_Z1 - SLOT_Z0 + 2 * SLOT_R, 2 * SLOT_R, angle=90)
    .extrude(UP_W + 2)
)

# shallow counter recess around the slot on the inner face of the left upright
cuts.append(
    cq.Workplane("YZ", origin=(XL + TAB_W, 0, 0))
    .center(Y_WC, SLOT_Z0 + 30)
    .slot2D(60 + 2 * LEDGE_R, 2 * LEDGE_R, angle=90)
    .extrude(UP_W - TAB_W + 1)
)

tool = cuts[0]
for c in cuts[1:]:
    tool = tool.union(c)
body = body.cut(tool)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
